import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 120.0          # plate width  (X)
H = 100.0          # plate height (Z)
T = 26.0           # plate thickness (Y); front face at -T/2, back face at +T/2
R_CORNER = 10.0    # rounding of the four plate corners (edges parallel to Y)

# back-side N-shaped guide channel
CH_W = 15.5                    # channel width
CH_DEPTH = 20.2                # channel depth measured from the back face
CH_ANG = 36.0                  # inclination of entry / exit legs (deg, rising toward -X)
L1U_ANG = 37.0                 # upper wall of the entry leg is slightly steeper
CH_Z0 = -10.0                  # channel centre height where it meets the side faces
LEG2_ANG = 16.0                # tilt of the middle leg from vertical (deg)
LEG2_X = -15.85                # middle-leg centre X at Z = LEG2_Z
LEG2_Z = 3.5
R_TIP = 5.0                    # tongue tip radius (inner side of hairpin)
R_HAIR = 22.0                  # outer radius of the hairpin bend
R_BOT_OUT = 21.0               # outer radius of the lower bend
R_BOT_IN = 6.0                 # inner radius of the lower bend
LOW_ANG = 33.0                 # lower wall of exit leg: inclination (deg)
LOW_P = (-43.5, -32.6)         # point on that lower wall
MOUTH_ANG = 10.0               # flattened lip at the exit mouth (deg)
MOUTH_Z = -25.0                # height where the lower lip meets the -X face
R_MOUTH = 20.0                 # blend between lower wall and lip
R_EXIT_UP = 20.0               # rounding where the exit leg meets the -X face (upper)
R_EXIT_LO = 1.5                # rounding where the lip meets the -X face

# through holes
HOLE_X = 9.3
HOLE_Z1 = -1.7
HOLE_Z2 = -39.05
HOLE_D = 5.0
CB_D = 9.0                     # counterbore diameter on the back face
CB_DEPTH = 3.5                 # counterbore depth

# front lightening pockets
P_DEPTH = 14.0                 # depth of the upper pockets (leaves a 12 mm back wall)
LR_R1 = 14.7                   # lower-right pocket: clearance radius around holes (front)
LR_R2 = 17.0                   # lower-right pocket: clearance radius (deep step)
LR_D1 = 10.5
LR_D2 = 14.0
LR_XR = 48.0                   # right edge of lower-right pocket
LR_ZB = -38.0                 # bottom edge of lower-right pocket
LR_TOP_X, LR_TOP_Z = 23.2, -7.1  # sloping top edge of lower-right pocket passes
LR_TOP_Z2 = -25.4                #   through (LR_TOP_X, LR_TOP_Z) and (LR_XR, LR_TOP_Z2)
TRI = [(29.0, 37.8), (48.2, 37.8), (48.2, 23.7)]   # triangular pocket (X, Z)
# upper-left pocket: left edge, top edge, concave arc, straight flank, sloped bottom, corner blend
UL_XL, UL_ZT = -47.9, 37.76
UL_ARC = [(-36.4, 37.76), (-40.25, 24.5), (-39.35, 16.1)]
UL_LOW = (-33.7, -5.1)
UL_BLEND = [(-43.7, 1.8), (-46.6, 4.9), (-47.9, 9.2)]

YF = -T / 2.0      # front face
YB = T / 2.0       # back face


# ---------------- helpers ----------------
def _norm(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def rounded_polygon(pts, radii):
    """For a closed polygon pts (x, z) return, per vertex, the tangent points and arc
    mid-point of a blend of radius radii[i] (0 = sharp corner)."""
    n = len(pts)
    corners = []
    for i in range(n):
        v = pts[i]
        r = radii[i]
        if r <= 0:
            corners.append((v, None, v))
            continue
        p = pts[i - 1]
        q = pts[(i + 1) % n]
        u1 = _norm((p[0] - v[0], p[1] - v[1]))
        u2 = _norm((q[0] - v[0], q[1] - v[1]))
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        half = math.acos(cosang) / 2.0
        t = r / math.tan(half)
        t1 = (v[0] + u1[0] * t, v[1] + u1[1] * t)
        t2 = (v[0] + u2[0] * t, v[1] + u2[1] * t)
        b = _norm((u1[0] + u2[0], u1[1] + u2[1]))
        dc = r / math.sin(half)
        c = (v[0] + b[0] * dc, v[1] + b[1] * dc)
        m = (c[0] - b[0] * r, c[1] - b[1] * r)
        corners.append((t1, m, t2))
    return corners


def profile_solid(pts, radii, y0, y1):
    """Prism in Y from y0 to y1 of a rounded polygon drawn in the XZ plane."""
    corners = rounded_polygon(pts, radii)
    wp = cq.Workplane(xz_plane(y0))
    L = Lz
    n = len(corners)
    start = corners[0][2]
    wp = wp.moveTo(*L(start))
    for i in range(1, n + 1):
        t1, m, t2 = corners[i % n]
        wp = wp.lineTo(*L(t1))
        if m is not None:
            wp = wp.threePointArc(L(m), L(t2))
    wp = wp.close()
    return wp.extrude(y1 - y0)


def xz_plane(y):
    # plane parallel to XZ at height y, normal +Y; its local y axis is -Z
    return cq.Plane(origin=(0, y, 0), xDir=(1, 0, 0), normal=(0, 1, 0))


def Lz(p):
    # model (X, Z) -> local coordinates of xz_plane
    return (p[0], -p[1])


def line_int(p1, d1, p2, d2):
    """Intersection of two 2D lines p + t d."""
    det = d1[0] * (-d2[1]) - d1[1] * (-d2[0])
    rx, rz = p2[0] - p1[0], p2[1] - p1[1]
    t = (rx * (-d2[1]) - rz * (-d2[0])) / det
    return (p1[0] + t * d1[0], p1[1] + t * d1[1])


# ---------------- base plate ----------------
plate = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(T / 2.0, both=True)
    .edges("|Y")
    .fillet(R_CORNER)
)

# ---------------- back channel ----------------
ta = math.tan(math.radians(CH_ANG))
hv = (CH_W / 2.0) / math.cos(math.radians(CH_ANG))     # vertical half extent of inclined legs
d1 = (-math.cos(math.radians(CH_ANG)), math.sin(math.radians(CH_ANG)))  # direction of inclined legs
k2 = math.radians(LEG2_ANG)
d2 = (math.sin(k2), -math.cos(k2))                      # middle leg direction (going down)
hh = (CH_W / 2.0) / math.cos(k2)                        # horizontal half extent of middle leg

d1u = (-math.cos(math.radians(L1U_ANG)), math.sin(math.radians(L1U_ANG)))
L1u = ((W / 2.0, CH_Z0 + hv), d1u)
L1l = ((W / 2.0, CH_Z0 - hv), d1)
L3u = ((-W / 2.0, CH_Z0 + hv), d1)
la = math.radians(LOW_ANG)
L3l = (LOW_P, (-math.cos(la), math.sin(la)))
ma = math.radians(MOUTH_ANG)
LMO = ((-W / 2.0, MOUTH_Z), (-math.cos(ma), math.sin(ma)))
L2i = ((LEG2_X + hh, LEG2_Z), d2)
L2o = ((LEG2_X - hh, LEG2_Z), d2)
LXM = ((-W / 2.0, 0.0), (0.0, 1.0))

XO = W / 2.0 + 12.0
v_start = (XO, CH_Z0 - hv - ta * 12.0)
v_tip = line_int(*L1l, *L2i)
v_bo = line_int(*L2i, *L3l)
v_mo = line_int(*L3l, *LMO)
v_xl = line_int(*LMO, *LXM)
v_out1 = (-W / 2.0, -H / 2.0 + 5.0)
v_out2 = (-W / 2.0 - 12.0, -H / 2.0 + 5.0)
v_out3 = (-W / 2.0 - 12.0, 30.0)
v_out4 = (-W / 2.0, 30.0)
v_xu = line_int(*L3u, *LXM)
v_bi = line_int(*L3u, *L2o)
v_ho = line_int(*L2o, *L1u)
v_end = (XO, CH_Z0 + hv - ta * 12.0)

ch_pts = [v_start, v_tip, v_bo, v_mo, v_xl, v_out1, v_out2, v_out3, v_out4, v_xu, v_bi, v_ho, v_end]
ch_r = [0, R_TIP, R_BOT_OUT, R_MOUTH, R_EXIT_LO, 0, 0, 0, 0, R_EXIT_UP, R_BOT_IN, R_HAIR, 0]
channel = profile_solid(ch_pts, ch_r, YB - CH_DEPTH, YB + 1.0)

part = plate.cut(channel)

# ---------------- front pockets ----------------
# triangle pocket
tri = profile_solid(TRI, [0, 0, 0], YF - 1.0, YF + P_DEPTH)
part = part.cut(tri)

# upper-left curved pocket (lines + arcs)
ul = (
    cq.Workplane(xz_plane(YF - 1.0))
    .moveTo(*Lz((UL_XL, UL_ZT)))
    .lineTo(*Lz(UL_ARC[0]))
    .threePointArc(Lz(UL_ARC[1]), Lz(UL_ARC[2]))
    .lineTo(*Lz(UL_LOW))
    .lineTo(*Lz(UL_BLEND[0]))
    .threePointArc(Lz(UL_BLEND[1]), Lz(UL_BLEND[2]))
    .close()
    .extrude(P_DEPTH + 1.0)
)
part = part.cut(ul)

# lower-right pocket, stepped, clearing circles around the two holes
sl = (LR_TOP_Z - LR_TOP_Z2) / (LR_TOP_X - LR_XR)
z_at_hole = LR_TOP_Z + sl * (HOLE_X - LR_TOP_X)
lr_poly = [(HOLE_X, LR_ZB), (LR_XR, LR_ZB), (LR_XR, LR_TOP_Z + sl * (LR_XR - LR_TOP_X)), (HOLE_X, z_at_hole)]


def lr_pocket(rclear, depth):
    body = profile_solid(lr_poly, [0, 0, 0, 0], YF - 1.0, YF + depth)
    for hz in (HOLE_Z1, HOLE_Z2):
        cyl = (
            cq.Workplane(xz_plane(YF - 2.0))
            .center(HOLE_X, -hz)
            .circle(rclear)
            .extrude(depth + 4.0)
        )
        body = body.cut(cyl)
    return body


part = part.cut(lr_pocket(LR_R1, LR_D1))
part = part.cut(lr_pocket(LR_R2, LR_D2))

# ---------------- through holes with back counterbore ----------------
for hz in (HOLE_Z1, HOLE_Z2):
    hole = (
        cq.Workplane(xz_plane(YF - 1.0))
        .center(HOLE_X, -hz)
        .circle(HOLE_D / 2.0)
        .extrude(T + 2.0)
    )
    part = part.cut(hole)
    cb = (
        cq.Workplane(xz_plane(YB - CB_DEPTH))
        .center(HOLE_X, -hz)
        .circle(CB_D / 2.0)
        .extrude(CB_DEPTH + 1.0)
    )
    part = part.cut(cb)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
